import cadquery as cq

# =====================================================================
# Enclosure base: rounded rectangular tray with a mating lip, two
# diagonal screw bosses, a PCB guide rib with a low tapered web, a thinned
# wall pocket with a window on the -X side and a window in the +Y wall.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
L = 120.0            # outer length (X)
W = 69.4             # outer width (Y)
H_body = 13.35       # outer body height up to the ledge
H_lip = 2.25         # height of the mating lip above the ledge
t_wall = 2.25        # total wall thickness
ledge = 1.5          # width of the ledge outside the lip
R_out = 3.3          # vertical outer corner radius
R_in = 1.0           # vertical inner corner radius
floor_t = 2.25       # floor thickness
bot_fillet = 1.0     # bottom outer edge round

# screw bosses (diagonal corners -X-Y and +X+Y)
boss_off = 9.6       # boss centre distance from the outer edges
boss_d = 10.8
boss_hole_d = 6.1
boss_top = 13.1      # z of the boss top
boss_hole_bottom = 3.5

# straight guide rib from the -X wall towards the middle (round end)
rib_y = -2.2         # rib centre line
rib_w = 1.5
rib_h = 1.75
rib_tip_x = 4.3      # x of the rounded tip

# low tapered web from the -X-Y boss to the rib tip
web_up = 0.8         # +Y edge offset from the boss centre (at boss centre x)
web_dn = 4.9         # -Y edge offset from the boss centre (at boss centre x)
web_h = 0.4          # height at the boss (falls to 0 at the tip)

# pocket thinning the inner face of the -X wall
rec_depth = 1.5
rec_top = 6.7
rec_gap = 0.4        # gap between rib and pocket start

# window through the -X wall (inside the pocket)
sx_yc = 15.0
sx_w = 9.3
sx_z0 = 2.35
sx_z1 = 5.6

# window through the +Y wall
sy_xc = 33.6
sy_w = 12.1
sy_z0 = 5.9
sy_z1 = 9.45

# ---------------- derived ----------------
H_tot = H_body + H_lip
xi = L / 2 - t_wall              # inner face |x|
yi = W / 2 - t_wall              # inner face |y|
bx = L / 2 - boss_off
by = W / 2 - boss_off
boss_pts = [(-bx, -by), (bx, by)]

# ---------------- outer shell ----------------
body = (
    cq.Workplane("XY")
    .box(L, W, H_body, centered=(True, True, False))
    .edges("|Z").fillet(R_out)
    .faces("<Z").edges().fillet(bot_fillet)
)
lip = (
    cq.Workplane("XY").workplane(offset=H_body - 0.01)
    .rect(L - 2 * ledge, W - 2 * ledge)
    .extrude(H_lip + 0.01)
    .edges("|Z").fillet(R_out - ledge)
)
shell = body.union(lip)

cavity = (
    cq.Workplane("XY").workplane(offset=floor_t)
    .rect(2 * xi, 2 * yi)
    .extrude(H_tot)
    .edges("|Z").fillet(R_in)
)
shell = shell.cut(cavity)

# ---------------- pocket on the inner -X wall ----------------
rec_y0 = rib_y + rib_w / 2.0 + rec_gap   # starts just past the rib
rec_y1 = yi - R_in               # ends at the inner corner round
recess = (
    cq.Workplane("XY")
    .box(rec_depth + 1.0, rec_y1 - rec_y0, rec_top - floor_t, centered=False)
    .translate((-xi - rec_depth, rec_y0, floor_t))
)
shell = shell.cut(recess)

# ---------------- windows ----------------
slot_x = (
    cq.Workplane("XY")
    .box(t_wall * 3, sx_w, sx_z1 - sx_z0)
    .translate((-L / 2, sx_yc, (sx_z0 + sx_z1) / 2))
)
slot_y = (
    cq.Workplane("XY")
    .box(sy_w, t_wall * 3, sy_z1 - sy_z0)
    .translate((sy_xc, W / 2, (sy_z0 + sy_z1) / 2))
)
shell = shell.cut(slot_x).cut(slot_y)

# ---------------- screw bosses ----------------
bosses = (
    cq.Workplane("XY").workplane(offset=floor_t - 0.01)
    .pushPoints(boss_pts)
    .circle(boss_d / 2)
    .extrude(boss_top - floor_t + 0.01)
)
shell = shell.union(bosses)

# ---------------- straight rib with round end ----------------
rib_x0 = -xi - 0.5
rib_xc = rib_tip_x - rib_w / 2.0
rib = (
    cq.Workplane("XY")
    .box(rib_xc - rib_x0, rib_w, rib_h + 0.01, centered=False)
    .translate((rib_x0, rib_y - rib_w / 2, floor_t - 0.01))
)
rib_end = (
    cq.Workplane("XY").workplane(offset=floor_t - 0.01)
    .center(rib_xc, rib_y).circle(rib_w / 2).extrude(rib_h + 0.01)
)
shell = shell.union(rib).union(rib_end)

# ---------------- low tapered web (boss -> rib tip) ----------------
tip = (rib_xc - 0.3, rib_y - rib_w / 2 - 0.2)
base_u = (-bx, -by + web_up)
base_d = (-bx, -by - web_dn)
web_plan = (
    cq.Workplane("XY").workplane(offset=floor_t - 0.01)
    .polyline([base_d, tip, base_u]).close()
    .extrude(web_h + 0.01)
)
# top of the web slopes linearly from web_h (boss centre) to 0 (tip)
web_prof = (
    cq.Workplane("XZ", origin=(0, 0, floor_t - 0.01))
    .polyline([
        (base_u[0] - 2.0, 0.0),
        (tip[0], 0.0),
        (tip[0], 0.01),
        (base_u[0], web_h + 0.01),
        (base_u[0] - 2.0, web_h + 0.01),
    ]).close()
    .extrude(40.0, both=True)
)
web = web_plan.intersect(web_prof)
shell = shell.union(web)

# ---------------- boss holes ----------------
holes = (
    cq.Workplane("XY").workplane(offset=boss_hole_bottom)
    .pushPoints(boss_pts)
    .circle(boss_hole_d / 2)
    .extrude(H_tot)
)
shell = shell.cut(holes)

result = shell
VIEW = {"azimuth": 45, "elevation": 26}
